import cadquery as cq

# =====================================================================
#  Mounting plate with a lobed opening, a wire groove and a fuse clip
#  (two bodies: the thick plate and the sheet-metal clip)
# =====================================================================

# ---------------- plate (mm) ----------------
W = 100.6          # plate width  (X)
L = 154.0          # plate length (Y)
T = 15.2           # plate thickness (Z)
RC = 29.5          # plan corner radius

# lobed opening = big central circle + two end lobes
R_BIG = 41.8
R_LOBE = 30.8
Y_LOBE = 25.3      # lobe centres at +/- Y_LOBE

# two through holes (diagonally opposite)
HOLE_D = 6.8
HOLES = [(-23.6, 65.4), (23.6, -62.4)]

# blind holes from the underside
BLIND_D = 9.0
BLIND_DEPTH = 6.0
BLINDS = [(-39.0, -37.5), (38.6, 41.2), (13.8, 66.1)]

# wire groove on the top face, from the -Y edge into the opening
G_LEFT = 9.0       # left wall X (parallel to Y)
G_RIGHT0 = 15.7    # right wall X at the outer edge
G_RIGHT1 = 15.3    # right wall X at the opening (slight taper)
GD = 4.1           # groove depth
NOTCH_Y = -56.4    # at the opening the groove drops through the plate
NOTCH_CH = 0.8     # slanted cut at the back-left corner of the notch

# underside recess that takes the clip base
CX0, CX1 = 3.4, 20.2   # clip base X range
R_Y0 = -75.5           # recess start (just inside the -Y edge)
CLIP_T = 0.4           # clip sheet thickness = recess depth
SQ = 8.5               # square window in the clip base
SQ_X, SQ_Y = 12.0, -65.5
RIV_D = 6.5            # blind rivet hole in the plate
RIV_DEPTH = 4.0

# ---------------- clip (fuse-clip) ----------------
XC = 12.0          # finger pair centre X
TAB_Y1 = -35.6     # +Y end of the clip base (inside the opening)
LIP_T = 0.6        # end-stop lip thickness (Y)
LIP_H = 4.7        # height of the folded clip body
FIN_W = 6.6        # finger width along Y
DECK_HOLE_D = 2.6  # pierced hole in the clip deck
DECK_HOLE_Y = -39.4
# section of the -X finger (dx from XC, z), rising from the clip deck: outer
# face up, rounded crest, concave gripping face back down
FIN_PTS = [(-6.8, 4.5), (-6.9, T - 6.7), (-7.1, T - 4.0), (-6.8, T - 1.55),
           (-5.8, T + 1.0), (-4.3, T + 2.1), (-3.3, T + 1.0), (-4.0, T - 0.6),
           (-4.5, T - 2.6), (-4.2, T - 4.6), (-2.8, T - 7.2), (-2.7, 6.2), (-2.9, 4.5)]


# ---------------- plate body ----------------
plate = (cq.Workplane("XY")
         .sketch().rect(W, L).vertices().fillet(RC).finalize()
         .extrude(T))

opening = (cq.Workplane("XY").workplane(offset=-1).circle(R_BIG).extrude(T + 2)
           .union(cq.Workplane("XY").workplane(offset=-1)
                  .pushPoints([(0, Y_LOBE), (0, -Y_LOBE)]).circle(R_LOBE).extrude(T + 2))
           .union(cq.Workplane("XY").workplane(offset=-1)
                  .rect(2 * R_LOBE, 2 * Y_LOBE).extrude(T + 2)))
plate = plate.cut(opening)

plate = plate.cut(cq.Workplane("XY").workplane(offset=-1)
                  .pushPoints(HOLES).circle(HOLE_D / 2).extrude(T + 2))

plate = plate.cut(cq.Workplane("XY").workplane(offset=-1)
                  .pushPoints(BLINDS).circle(BLIND_D / 2).extrude(BLIND_DEPTH + 1))


def _g_right(y):
    return G_RIGHT0 + (y + L / 2) * (G_RIGHT1 - G_RIGHT0) / (NOTCH_Y + L / 2)


def _groove_prism(y0, y1, z0, h):
    pts = [(G_LEFT, y0), (_g_right(y0), y0), (_g_right(y1), y1), (G_LEFT, y1)]
    return cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(h)


plate = plate.cut(_groove_prism(-L / 2 - 2, NOTCH_Y + 1, T - GD, GD + 1))
# wire notch: same walls as the groove, its back-left corner cut on a slant
notch_pts = [(G_LEFT, NOTCH_Y), (_g_right(NOTCH_Y), NOTCH_Y),
             (_g_right(NOTCH_Y + 12), NOTCH_Y + 12), (G_LEFT - NOTCH_CH * 1.7, NOTCH_Y + 12),
             (G_LEFT - NOTCH_CH * 1.7, NOTCH_Y + NOTCH_CH * 3.0)]
plate = plate.cut(cq.Workplane("XY").workplane(offset=-1)
                  .polyline(notch_pts).close().extrude(T + 2))

# underside recess for the clip base (runs out into the opening)
rec_len = 30.0
plate = plate.cut(cq.Workplane("XY").workplane(offset=-1)
                  .center((CX0 + CX1) / 2, R_Y0 + rec_len / 2)
                  .rect(CX1 - CX0, rec_len).extrude(CLIP_T + 1))
# blind rivet hole above the clip window
plate = plate.cut(cq.Workplane("XY").workplane(offset=-1)
                  .center(SQ_X, SQ_Y).circle(RIV_D / 2).extrude(RIV_DEPTH + 1))

# ---------------- clip body ----------------
base_len = TAB_Y1 - R_Y0
clip = (cq.Workplane("XY")
        .center((CX0 + CX1) / 2, R_Y0 + base_len / 2)
        .rect(CX1 - CX0, base_len).extrude(CLIP_T))
# square window in the base under the rivet hole
clip = clip.cut(cq.Workplane("XY").workplane(offset=-1)
                .center(SQ_X, SQ_Y).rect(SQ, SQ).extrude(CLIP_T + 2))
# folded end wall
clip = clip.union(cq.Workplane("XY")
                  .center((CX0 + CX1) / 2, TAB_Y1 - LIP_T / 2)
                  .rect(CX1 - CX0, LIP_T).extrude(LIP_H))
# folded-back upper deck carrying the fingers; it runs back to the opening wall
# (and into the wire notch), so it is trimmed by the plate itself
deck_y0 = NOTCH_Y - 2.0
deck = (cq.Workplane("XY").workplane(offset=LIP_H - CLIP_T)
        .center((CX0 + CX1) / 2, (deck_y0 + TAB_Y1) / 2)
        .rect(CX1 - CX0, TAB_Y1 - deck_y0).extrude(CLIP_T))
deck = deck.cut(plate)
# small pierced hole in the deck between the fingers
deck = deck.cut(cq.Workplane("XY").workplane(offset=LIP_H - CLIP_T - 1)
                .center(XC, DECK_HOLE_Y).circle(DECK_HOLE_D / 2).extrude(CLIP_T + 2))
clip = clip.union(deck)


def finger(sign):
    pts = [(XC + sign * dx, z) for dx, z in FIN_PTS]
    prof = (cq.Workplane("XZ", origin=(0, TAB_Y1 - LIP_T, 0))
            .moveTo(*pts[0])
            .spline(pts[1:], includeCurrent=True)
            .close())
    return prof.extrude(FIN_W)


clip = clip.union(finger(1)).union(finger(-1))

result = cq.Workplane("XY").add(plate.solids().vals()).add(clip.solids().vals())

VIEW = {"azimuth": 45, "elevation": 26}
